import math
import cadquery as cq

# =====================================================================
# Hose-barb reducer: tapered socket body -> 45 deg shoulder -> neck ->
# three sharp-stepped barbs.  Axis of revolution = X axis, socket end
# at -X, barb tip at +X.  All dimensions in millimetres.
# =====================================================================

# ---------------- driving dimensions ----------------
BODY_LEN = 30.5           # tapered socket body length
BODY_R_OPEN = 17.7        # outer radius at the open (socket) end
BODY_R_SHOULDER = 19.35   # outer radius at the shoulder (cone start)
CONE_LEN = 8.5            # conical shoulder length
NECK_R = 10.85            # neck radius (end of shoulder cone)
NECK_LEN = 5.1            # plain neck before the first barb
BARB_COUNT = 3
BARB_LEN = 9.0            # axial length of each barb
BARB_R_MAX = 12.1         # barb crest radius (sharp step side)
BARB_R_MIN = 10.95        # barb radius at its tapered (tip-side) end
BORE_R = 8.1              # through-bore radius
SOCKET_R = 12.7           # socket bore radius
SOCKET_DEPTH = 17.0       # depth of the cylindrical socket from the open end
SOCKET_CONE_ANGLE = 45.0  # socket bottom cone: angle between cone and axis (deg)

# angular position (about X, from +Y toward +Z) of the revolve seams;
# purely cosmetic - they keep the seam edges out of the standard views
SEAM_BODY = -50.4
SEAM_SHOULDER = 0.0
SEAM_BARBS = -44.3
SEAM_SOCKET = 34.6
SEAM_BORE = 185.0

# ---------------- derived stations along X ----------------
x0 = 0.0
x_sh = x0 + BODY_LEN
x_cone = x_sh + CONE_LEN
x_neck = x_cone + NECK_LEN
x_tip = x_neck + BARB_COUNT * BARB_LEN
x_mid = 0.5 * (x0 + x_tip)          # centre the part on the origin
sock_cone_len = (SOCKET_R - BORE_R) / math.tan(math.radians(SOCKET_CONE_ANGLE))
x_sock_end = x0 + SOCKET_DEPTH + sock_cone_len


def revolved(profile, seam_deg):
    """Revolve a closed (x, r) profile about the X axis; rotate the seam."""
    pts = [(px - x_mid, pr) for px, pr in profile]
    solid = (
        cq.Workplane("XY")
        .polyline(pts)
        .close()
        .revolve(360.0, (0, 0, 0), (1, 0, 0))
    )
    return solid.rotate((0, 0, 0), (1, 0, 0), seam_deg)


# ---------------- outer body ----------------
body = revolved(
    [(x0, 0), (x0, BODY_R_OPEN), (x_sh, BODY_R_SHOULDER), (x_sh, 0)], SEAM_BODY
)
shoulder = revolved(
    [(x_sh, 0), (x_sh, BODY_R_SHOULDER), (x_cone, NECK_R), (x_cone, 0)], SEAM_SHOULDER
)

barb_prof = [(x_cone, 0), (x_cone, NECK_R), (x_neck, NECK_R)]
xb = x_neck
for i in range(BARB_COUNT):
    barb_prof.append((xb, BARB_R_MAX))       # sharp retaining step
    xb += BARB_LEN
    barb_prof.append((xb, BARB_R_MIN))       # taper toward the tip
barb_prof.append((x_tip, 0))
barbs = revolved(barb_prof, SEAM_BARBS)

outer = body.union(shoulder).union(barbs)

# ---------------- internal passages ----------------
socket = revolved(
    [
        (x0 - 1.0, 0),
        (x0 - 1.0, SOCKET_R),
        (x0 + SOCKET_DEPTH, SOCKET_R),
        (x_sock_end, BORE_R),
        (x_sock_end, 0),
    ],
    SEAM_SOCKET,
)
bore = revolved(
    [
        (x_sock_end - 1.0, 0),
        (x_sock_end - 1.0, BORE_R),
        (x_tip + 1.0, BORE_R),
        (x_tip + 1.0, 0),
    ],
    SEAM_BORE,
)

result = outer.cut(socket).cut(bore)

VIEW = {"azimuth": 45, "elevation": 26}
